import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 200.0            # plate length (X)
W = 100.0            # plate width (Y)
R_CORNER = 12.0      # outer corner radius (plan view)
H = 7.6              # overall plate height (top of rim)

RIM_W = 2.5          # width of the raised rim
POCKET_D = 2.8       # depth of top recess below rim top
POCKET_FILLET = 0.0  # fillet at the floor of the top recess (0 = sharp)

BOT_RING_W = 2.5     # width of the bottom contact ring
BOT_RECESS_D = 0.6   # depth of the shallow recess on the underside

BOSS_X = 66.4        # boss centre X
BOSS_BX = 42.6       # boss base size X (at the recess floor)
BOSS_BY = 49.8       # boss base size Y
BOSS_TX = 30.0       # boss top size X
BOSS_TY = 37.8       # boss top size Y
BOSS_TOP_ABOVE_RIM = 3.7

HOLE_D = 8.0         # through hole
HOLE_PITCH = 18.8    # hole spacing along Y
CSK_D = 18.0         # countersink diameter on the underside
CSK_ANGLE = 90.0

floor_z = H - POCKET_D
boss_h = H + BOSS_TOP_ABOVE_RIM - floor_z

# ---------------- base plate ----------------
plate = (cq.Workplane("XY")
         .rect(L, W)
         .extrude(H)
         .edges("|Z").fillet(R_CORNER))

# top recess inside the rim
pocket = (cq.Workplane("XY").workplane(offset=floor_z)
          .rect(L - 2 * RIM_W, W - 2 * RIM_W)
          .extrude(POCKET_D + 1.0)
          .edges("|Z").fillet(R_CORNER - RIM_W))
plate = plate.cut(pocket)
if POCKET_FILLET > 0:
    plate = (plate.faces(cq.selectors.NearestToPointSelector((0, 0, floor_z)))
             .edges().fillet(POCKET_FILLET))

# shallow recess on the underside, leaving a narrow contact ring
bot = (cq.Workplane("XY").workplane(offset=-1.0)
       .rect(L - 2 * BOT_RING_W, W - 2 * BOT_RING_W)
       .extrude(1.0 + BOT_RECESS_D)
       .edges("|Z").fillet(R_CORNER - BOT_RING_W))
plate = plate.cut(bot)

# ---------------- tapered boss (truncated pyramid, planar faces) ----------------
def frustum(cx, cy, z0, bx, by, tx, ty, h):
    V = cq.Vector
    b = [V(cx - bx / 2, cy - by / 2, z0), V(cx + bx / 2, cy - by / 2, z0),
         V(cx + bx / 2, cy + by / 2, z0), V(cx - bx / 2, cy + by / 2, z0)]
    t = [V(cx - tx / 2, cy - ty / 2, z0 + h), V(cx + tx / 2, cy - ty / 2, z0 + h),
         V(cx + tx / 2, cy + ty / 2, z0 + h), V(cx - tx / 2, cy + ty / 2, z0 + h)]
    faces = [cq.Face.makeFromWires(cq.Wire.makePolygon(b[::-1], close=True)),
             cq.Face.makeFromWires(cq.Wire.makePolygon(t, close=True))]
    for i in range(4):
        j = (i + 1) % 4
        faces.append(cq.Face.makeFromWires(
            cq.Wire.makePolygon([b[i], b[j], t[j], t[i]], close=True)))
    return cq.Solid.makeSolid(cq.Shell.makeShell(faces)).fix()

# start slightly below the floor so the union is clean
boss = frustum(BOSS_X, 0.0, floor_z - 0.5,
               BOSS_BX + (BOSS_BX - BOSS_TX) * 0.5 / boss_h,
               BOSS_BY + (BOSS_BY - BOSS_TY) * 0.5 / boss_h,
               BOSS_TX, BOSS_TY, boss_h + 0.5)
plate = plate.union(cq.Workplane("XY").add(boss))

# ---------------- through holes, countersunk from below ----------------
tan_half = math.tan(math.radians(CSK_ANGLE / 2.0))
csk_z0 = BOT_RECESS_D - 1.0          # start the cone 1 mm below the underside face
for yy in (-HOLE_PITCH / 2.0, HOLE_PITCH / 2.0):
    drill = (cq.Workplane("XY").workplane(offset=-1.0)
             .center(BOSS_X, yy)
             .circle(HOLE_D / 2.0)
             .extrude(H + BOSS_TOP_ABOVE_RIM + 2.0))
    cone = cq.Solid.makeCone(CSK_D / 2.0 + 1.0 * tan_half,        # radius at csk_z0
                             0.0,                                   # apex
                             CSK_D / 2.0 / tan_half + 1.0,          # height to apex
                             pnt=cq.Vector(BOSS_X, yy, csk_z0),
                             dir=cq.Vector(0, 0, 1))
    plate = plate.cut(drill).cut(cq.Workplane("XY").add(cone))

result = plate

VIEW = {"azimuth": 45, "elevation": 26}
